import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BODY = 100.0          # cube body edge length (X, Y, Z)
RAIL_W = 8.5          # square section of frame members and rails
RAIL_EXT = 6.3        # rail protrusion beyond the front and back faces (along Y)
RAIL_R = 1.2          # rounding of rail long edges
END_R = 1.0           # rounding of rail end faces
PANEL_T = 3.0         # panel plate thickness (panels sit flush in the frame)
HOLE_OFF = 39.0       # hole centre distance from face centre
HOLE_D = 2.8          # panel hole diameter

H = BODY / 2.0
OPEN = BODY - 2 * RAIL_W          # face opening / panel size
C = H - RAIL_W / 2.0              # centre line of an edge member


def box(sx, sy, sz, cx=0.0, cy=0.0, cz=0.0):
    return cq.Workplane("XY").box(sx, sy, sz).translate((cx, cy, cz))


def rail(sx, sz):
    """Rail along Y at corner (sx, sz): rounded outer edge over the full length,
    fully rounded stand-off ends protruding from the front and back faces."""
    mid = cq.Workplane("XY").box(RAIL_W, BODY, RAIL_W)
    mid = mid.edges("|Y").edges(
        cq.selectors.NearestToPointSelector((sx * RAIL_W, 0, sz * RAIL_W))
    ).fillet(RAIL_R)
    r = mid
    for sy in (-1, 1):
        end = (
            cq.Workplane("XZ", origin=(0, sy * H, 0))
            .rect(RAIL_W, RAIL_W)
            .extrude(-sy * RAIL_EXT)
            .edges("|Y")
            .fillet(RAIL_R)
        )
        end = end.faces(">Y" if sy > 0 else "<Y").edges().fillet(END_R)
        r = r.union(end)
    return r.translate((sx * C, 0, sz * C))


# ---------------- frame ----------------
frame = None
for sx in (-1, 1):
    for sz in (-1, 1):
        rl = rail(sx, sz)
        frame = rl if frame is None else frame.union(rl)

# cross members along X (front/back, top/bottom) between the rails
for sy in (-1, 1):
    for sz in (-1, 1):
        frame = frame.union(box(OPEN, RAIL_W, RAIL_W, cy=sy * C, cz=sz * C))

# vertical members along Z at the four XY corners between the rails
for sx in (-1, 1):
    for sy in (-1, 1):
        frame = frame.union(box(RAIL_W, RAIL_W, OPEN, cx=sx * C, cy=sy * C))

# ---------------- flush panels with four screw holes each ----------------
pc = H - PANEL_T / 2.0
hole_pts = [(0, HOLE_OFF), (0, -HOLE_OFF), (HOLE_OFF, 0), (-HOLE_OFF, 0)]


def panel(normal_axis, sign):
    if normal_axis == "X":
        wp = cq.Workplane("YZ", origin=(sign * pc, 0, 0))
    elif normal_axis == "Y":
        wp = cq.Workplane("XZ", origin=(0, sign * pc, 0))
    else:
        wp = cq.Workplane("XY", origin=(0, 0, sign * pc))
    p = wp.rect(OPEN, OPEN).extrude(PANEL_T / 2.0, both=True)
    holes = wp.pushPoints(hole_pts).circle(HOLE_D / 2.0).extrude(PANEL_T, both=True)
    return p.cut(holes)


parts = [frame.val()]
for ax in ("X", "Y", "Z"):
    for s in (-1, 1):
        parts.append(panel(ax, s).val())

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(parts)])

VIEW = {"azimuth": 45, "elevation": 26}
